import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
W = 100.0          # overall width along Y (top band incl. tabs)
H = 33.4           # overall height along Z
T = 1.6            # plate thickness along X
TAB_OVER = 4.2     # overhang of top band beyond the lower body, each side
TAB_H = 6.5        # height of the top band

# relief heights (raised on the +X face)
H_BIG = 0.9        # logo + "BOSCH"
H_SMALL = 0.4      # two lower text lines

FONT_NAME = "DejaVu Sans"
FONT_BOLD = "bold"
FONT_REG = "regular"
ROUND_DOTS = True  # the i-dots of the lettering are round
DOT_SCALE = 1.0    # dot diameter relative to the font's square dot

# text lines fitted into boxes on the +X face:
# (text, font, y_min, y_max, z_min, z_max, relief height, glyph width gain)
# y measured along +Y from the plate centre, z along +Z from the plate centre
TEXTS = [
    ("BOSCH", FONT_BOLD, -8.2, 24.2, 5.62, 12.98, H_BIG, 1.07),
    ("Winkelschleifer", FONT_BOLD, -31.75, 31.3, -4.4, 2.1, H_SMALL, 1.0),
    ("GWX 18V-15 SC", FONT_REG, -26.3, 26.25, -13.42, -8.32, H_SMALL, 1.1),
]

# Bosch armature logo
LOGO_Y = -18.7
LOGO_Z = 9.26
R_OUT = 5.35        # ring outer radius
R_RING_IN = 4.8     # ring inner radius
R_ARC_OUT = 4.0     # D-arc outer radius
R_ARC_IN = 3.45     # D-arc inner radius
BAR_U0 = 1.75       # vertical bars inner offset from logo centre
BAR_U1 = 2.25       # vertical bars outer offset
XBAR_V0 = 0.95      # horizontal bars inner offset
XBAR_V1 = 1.45      # horizontal bars outer offset

# ---------------- base plate ----------------
body_w = W - 2 * TAB_OVER
plate = (
    cq.Workplane("YZ")
    .polyline([
        (-body_w / 2, -H / 2),
        (body_w / 2, -H / 2),
        (body_w / 2, H / 2 - TAB_H),
        (W / 2, H / 2 - TAB_H),
        (W / 2, H / 2),
        (-W / 2, H / 2),
        (-W / 2, H / 2 - TAB_H),
        (-body_w / 2, H / 2 - TAB_H),
    ])
    .close()
    .extrude(T)
)

# face workplane on the +X side (local x = +Y, local y = +Z)
def face_wp():
    return cq.Workplane("YZ", origin=(T, 0, 0))


# ---------------- raised lettering ----------------
def _letter_groups(solids):
    """Group solids of a text compound into glyphs (e.g. 'i' = stem + dot)."""
    items = sorted(solids, key=lambda so: so.BoundingBox().ymin)
    groups = []
    for so in items:
        bb = so.BoundingBox()
        if groups:
            g = groups[-1]
            ov = min(g["y1"], bb.ymax) - max(g["y0"], bb.ymin)
            if ov > 0.5 * min(g["y1"] - g["y0"], bb.ymax - bb.ymin):
                g["solids"].append(so)
                g["y0"] = min(g["y0"], bb.ymin)
                g["y1"] = max(g["y1"], bb.ymax)
                continue
        groups.append({"solids": [so], "y0": bb.ymin, "y1": bb.ymax})
    return groups


def fitted_text(txt, font, y0, y1, z0, z1, h, glyph_gain=1.0):
    """Raised lettering scaled to fill the box [y0,y1] x [z0,z1].

    glyph_gain > 1 widens every glyph about its own centre relative to the
    letter pitch (tighter tracking)."""
    t = face_wp().text(txt, 10.0, h, font=FONT_NAME, kind=font,
                       halign="center", valign="center").val()
    bb = t.BoundingBox()
    groups = _letter_groups(t.Solids())
    # extents after widening each glyph about its centre
    ys = []
    for g in groups:
        c = 0.5 * (g["y0"] + g["y1"])
        ys += [c + glyph_gain * (g["y0"] - c), c + glyph_gain * (g["y1"] - c)]
    Y0, Y1 = min(ys), max(ys)
    sy = (y1 - y0) / (Y1 - Y0)
    sz = (z1 - z0) / bb.zlen
    out = []
    for g in groups:
        c = 0.5 * (g["y0"] + g["y1"])
        m = cq.Matrix([
            [1, 0, 0, 0],
            [0, sy * glyph_gain, 0, sy * (c * (1 - glyph_gain) - Y0) + y0],
            [0, 0, sz, z0 - sz * bb.zmin],
        ])
        parts = [so.transformGeometry(m) for so in g["solids"]]
        if ROUND_DOTS and len(parts) == 2:
            # i-dot: replace the upper (smaller) piece by a round dot
            parts.sort(key=lambda p: p.BoundingBox().zmin)
            dbb = parts[1].BoundingBox()
            d = DOT_SCALE * min(dbb.ylen, dbb.zlen)
            dot = (
                face_wp()
                .center(0.5 * (dbb.ymin + dbb.ymax), 0.5 * (dbb.zmin + dbb.zmax))
                .circle(d / 2)
                .extrude(h)
                .val()
            )
            parts[1] = dot
        out += parts
    return cq.Compound.makeCompound(out)


result = plate
for txt, font, y0, y1, z0, z1, h, gain in TEXTS:
    result = result.union(cq.Workplane().add(fitted_text(txt, font, y0, y1, z0, z1, h, gain)))

# ---------------- logo ----------------
def logo_solid(h):
    wp = face_wp().center(LOGO_Y, LOGO_Z)
    ring = wp.circle(R_OUT).circle(R_RING_IN).extrude(h)
    arcs = face_wp().center(LOGO_Y, LOGO_Z).circle(R_ARC_OUT).circle(R_ARC_IN).extrude(h)
    # keep only the side parts of the arc ring (|u| >= BAR_U1)
    keep = (
        face_wp().center(LOGO_Y, LOGO_Z)
        .pushPoints([(-(BAR_U1 + 5), 0), ((BAR_U1 + 5), 0)])
        .rect(10, 12)
        .extrude(h)
    )
    arcs = arcs.intersect(keep)
    v_top = math.sqrt(R_ARC_OUT ** 2 - BAR_U1 ** 2)
    bars = (
        face_wp().center(LOGO_Y, LOGO_Z)
        .pushPoints([(-(BAR_U0 + BAR_U1) / 2, 0), ((BAR_U0 + BAR_U1) / 2, 0)])
        .rect(BAR_U1 - BAR_U0, 2 * v_top)
        .extrude(h)
    )
    xbars = (
        face_wp().center(LOGO_Y, LOGO_Z)
        .pushPoints([(0, (XBAR_V0 + XBAR_V1) / 2), (0, -(XBAR_V0 + XBAR_V1) / 2)])
        .rect(2 * BAR_U0 + 0.1, XBAR_V1 - XBAR_V0)
        .extrude(h)
    )
    return ring.union(arcs).union(bars).union(xbars)


result = result.union(logo_solid(H_BIG))
